import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
DISK_D = 100.0          # outer diameter of both discs
DISK_T = 11.0           # disc thickness
SPACING = 115.0         # centre distance between the two discs (along X)
SEAM_ANGLE = 45.0       # where the cylinder seam of each disc sits (cosmetic only)

# female disc (pentagon socket, 6 small holes) at -X
F_HOLE_D = 7.5
F_HOLE_PCD_R = 36.8
F_HOLE_N = 6
F_CBORE_D = 48.4
F_CBORE_DEPTH = 5.5
PENT_R = 20.0           # pentagon circumradius (socket and boss)

# male disc (pentagon boss, 3 large holes) at +X
M_HOLE_D = 14.0
M_HOLE_PCD_R = 34.0
M_HOLE_N = 3
BOSS_H = 10.7
BOSS_BORE_D = 24.2

def pentagon_pts(r, rot_deg=0.0):
    return [(r * math.cos(math.radians(rot_deg + 72 * i)),
             r * math.sin(math.radians(rot_deg + 72 * i))) for i in range(5)]

# ---------------- female disc ----------------
fx = -SPACING / 2.0
female = (cq.Workplane("XY").circle(DISK_D / 2).extrude(DISK_T)
          .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE).translate((fx, 0, 0)))
# counterbore
female = female.cut(
    cq.Workplane("XY").workplane(offset=DISK_T - F_CBORE_DEPTH)
    .center(fx, 0).circle(F_CBORE_D / 2).extrude(F_CBORE_DEPTH + 1))
# pentagon through socket
female = female.cut(
    cq.Workplane("XY").workplane(offset=-1).center(fx, 0)
    .polyline(pentagon_pts(PENT_R)).close().extrude(DISK_T + 2))
# bolt holes
f_holes = [(fx + F_HOLE_PCD_R * math.cos(math.radians(360.0 / F_HOLE_N * i)),
            F_HOLE_PCD_R * math.sin(math.radians(360.0 / F_HOLE_N * i)))
           for i in range(F_HOLE_N)]
female = female.cut(
    cq.Workplane("XY").workplane(offset=-1).pushPoints(f_holes)
    .circle(F_HOLE_D / 2).extrude(DISK_T + 2))

# ---------------- male disc ----------------
mx = SPACING / 2.0
male = (cq.Workplane("XY").circle(DISK_D / 2).extrude(DISK_T)
        .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE).translate((mx, 0, 0)))
boss = (cq.Workplane("XY").workplane(offset=DISK_T).center(mx, 0)
        .polyline(pentagon_pts(PENT_R)).close().extrude(BOSS_H))
male = male.union(boss)
male = male.cut(
    cq.Workplane("XY").workplane(offset=-1).center(mx, 0)
    .circle(BOSS_BORE_D / 2).extrude(DISK_T + BOSS_H + 2))
m_holes = [(mx + M_HOLE_PCD_R * math.cos(math.radians(360.0 / M_HOLE_N * i)),
            M_HOLE_PCD_R * math.sin(math.radians(360.0 / M_HOLE_N * i)))
           for i in range(M_HOLE_N)]
male = male.cut(
    cq.Workplane("XY").workplane(offset=-1).pushPoints(m_holes)
    .circle(M_HOLE_D / 2).extrude(DISK_T + 2))

result = female.union(male)

VIEW = {"azimuth": 45, "elevation": 26}
